import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Contact-carrier plate.
# The plate lies in the XZ plane: front face at Y=0, body extends to +Y,
# blocks / latch ears protrude from the front face toward -Y.
# ---------------------------------------------------------------------------

# overall plate
T = 3.0            # plate thickness (Y)
H = 62.2           # overall height (Z)
W_N = 14.8         # width of the narrow spine
W_W = 24.4         # width of the middle cross and of the lower wing section

# middle cross
Z_C = 42.2         # centre height of the middle cross (and of the central slot)
H_C = 11.6         # height of the middle cross

# lower wing section
Z_L = 12.27        # centre height of the lower wing section
H_L = 11.68        # its height

# top hole (through, counterbored from the back)
TOP_HOLE_D = 2.1
TOP_HOLE_Z = H - 2.15
TOP_CB_D = 3.2
CB_DEPTH = 1.0

# pockets in the front face (symmetric about Z_C)
P_W = 12.6         # pocket width
P_IN = 6.77        # distance from Z_C to the inner pocket edge
P_OUT = 15.7       # distance from Z_C to the outer pocket edge
P_D = 2.35         # pocket depth

# hairline grooves on the back along the pocket walls
BG_W = 0.12
BG_D = 0.15
BG_MARGIN = 1.3

# bowls (round recesses between the pockets and the slot)
BOWL_R = 5.3
BOWL_OFF = 8.63    # offset of the bowl centre from Z_C
BOWL_D = 1.7

# central slot (through) + conical relief from the back
SLOT_W = 5.5
SLOT_H = 10.0
SLOT_LIP = 1.1     # thickness of the front lip around the slot
SLOT_CB_R0 = 4.2   # relief radius at the lip
SLOT_CB_R1 = 4.85  # relief radius at the back face

# side holes in the cross arms (through, counterbored from the back)
SIDE_HOLE_X = 6.71
SIDE_HOLE_D = 2.2
SIDE_CB_D = 3.0

# square blocks protruding from the front face
BLK = 3.13         # block size in X and Z
BLK_P = 3.15       # protrusion in -Y

# pin channels in the cross arms (half-round grooves in the front face)
G_DZ = 3.53        # channel offset from Z_C
G_R = 1.16         # channel radius
G_END = 4.33       # |x| where the cylindrical part ends
G_TIP = 2.55       # |x| of the (closed) conical end next to the slot
G_TIP_R = 0.45     # radius at the conical end
RIB_X = (10.95, 8.0)   # |x| of the crush ribs at the channel rims
RIB_D = 0.28       # rib height (narrowing of the channel opening)
RIB_HW = 0.3       # rib half width (X)
RIB_T = 0.8        # rib depth (Y) behind the front face (clipped by the channel)

# latch ears (D-shaped bosses just outside the outer pocket ends)
EAR_R = 2.09       # radius of the D-shaped boss
EAR_YC = 0.46      # boss axis behind the front face (protrusion = R - YC)
EAR_X = 4.22       # ear centre |x|
EAR_OUT = 1.4      # height of the D boss
PIP_R0 = 1.5       # tapered round pip on the pocket-facing side of each ear
PIP_R1 = 1.15      # (base radius at the ear, end radius, height)
PIP_H = 0.5

# moulding windows behind the pips (through the pocket floor)
WIN_W = 2.3
WIN_Z0 = 0.15      # window spans edge -/+ (WIN_Z0 .. WIN_Z1)
WIN_Z1 = 0.45

# big lower opening (horizontal stadium)
OV_W = 14.7
OV_H = 11.62

# engraved marking "C+ 4" (glyphs placed individually: char, size, left x, base z)
TXT_BASE_Z = 21.27
TXT_SIZE = 4.0
TXT_DEPTH = 0.3
TXT_FONT = "DejaVu Serif"
TXT_GLYPHS = (("C", TXT_SIZE, -4.095, TXT_BASE_Z),
              ("+", 0.75 * TXT_SIZE, -1.50, TXT_BASE_Z + 0.52),
              ("4", TXT_SIZE, 1.527, TXT_BASE_Z))


# ------------------------------------------------------------------ helpers
def box(x0, x1, y0, y1, z0, z1):
    return cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0,
                            pnt=cq.Vector(x0, y0, z0))


def cyl_y(x, z, r, y0, y1):
    """cylinder with its axis along +Y from y0 to y1"""
    return cq.Solid.makeCylinder(r, y1 - y0, pnt=cq.Vector(x, y0, z),
                                 dir=cq.Vector(0, 1, 0))


def solid_of(wp):
    return wp.val()


# ------------------------------------------------------------------ base plate
zc0, zc1 = Z_C - H_C / 2, Z_C + H_C / 2
zl0, zl1 = Z_L - H_L / 2, Z_L + H_L / 2
n, w = W_N / 2, W_W / 2
outline = [(-n, 0), (n, 0), (n, zl0), (w, zl0), (w, zl1), (n, zl1),
           (n, zc0), (w, zc0), (w, zc1), (n, zc1), (n, H), (-n, H),
           (-n, zc1), (-w, zc1), (-w, zc0), (-n, zc0), (-n, zl1), (-w, zl1),
           (-w, zl0), (-n, zl0)]
plate = cq.Workplane("XZ").polyline(outline).close().extrude(-T).val()

# ------------------------------------------------------------------ first set of cuts
cuts = []

# pockets + hairline grooves on the back
for s in (1, -1):
    za, zb = sorted((Z_C + s * P_IN, Z_C + s * P_OUT))
    cuts.append(box(-P_W / 2, P_W / 2, -1, P_D, za, zb))
    for sx in (1, -1):
        xw = sx * P_W / 2
        cuts.append(box(xw - BG_W / 2, xw + BG_W / 2, T - BG_D, T + 1,
                        za + BG_MARGIN, zb - BG_MARGIN))

# bowls
for s in (1, -1):
    cuts.append(cyl_y(0, Z_C + s * BOWL_OFF, BOWL_R, -1, BOWL_D))

# central slot and its conical relief from the back
cuts.append(solid_of(cq.Workplane("XZ", origin=(0, 1, 0)).center(0, Z_C)
                     .slot2D(SLOT_H, SLOT_W, angle=90).extrude(-(T + 2))
                     .translate((0, -2, 0))))
_h = T - SLOT_LIP
_ext = 0.5
cuts.append(cq.Solid.makeCone(SLOT_CB_R0,
                              SLOT_CB_R1 + (SLOT_CB_R1 - SLOT_CB_R0) * _ext / _h,
                              _h + _ext, pnt=cq.Vector(0, SLOT_LIP, Z_C),
                              dir=cq.Vector(0, 1, 0)))

# top hole and side holes, each counterbored from the back
cuts.append(cyl_y(0, TOP_HOLE_Z, TOP_HOLE_D / 2, -1, T + 1))
cuts.append(cyl_y(0, TOP_HOLE_Z, TOP_CB_D / 2, T - CB_DEPTH, T + 1))
for s in (1, -1):
    cuts.append(cyl_y(s * SIDE_HOLE_X, Z_C, SIDE_HOLE_D / 2, -1, T + 1))
    cuts.append(cyl_y(s * SIDE_HOLE_X, Z_C, SIDE_CB_D / 2, T - CB_DEPTH, T + 1))

# pin channels: one revolved profile (conical inner end, open outer end)
x_out = W_W / 2 + 1.0
prof = [(G_TIP, 0.0), (G_TIP, G_TIP_R), (G_END, G_R),
        (x_out, G_R), (x_out, 0.0)]
chan_r = (cq.Workplane("XY").polyline(prof).close()
          .revolve(360, (0, 0, 0), (1, 0, 0)))
chan_l = chan_r.mirror("YZ")
for sz in (1, -1):
    zg = Z_C + sz * G_DZ
    cuts.append(chan_r.translate((0, 0, zg)).val())
    cuts.append(chan_l.translate((0, 0, zg)).val())

# big lower opening
cuts.append(solid_of(cq.Workplane("XZ", origin=(0, 1, 0)).center(0, Z_L)
                     .slot2D(OV_W, OV_H, angle=0).extrude(-(T + 2))
                     .translate((0, -2, 0))))

body = plate.cut(*cuts)

# ------------------------------------------------------------------ additions
adds = []

# square blocks on the cross arms and at the corners of the lower wings
for sx in (1, -1):
    xa, xb = sorted((sx * (w - BLK), sx * w))
    for za, zb in ((Z_C - BLK / 2, Z_C + BLK / 2),
                   (zl0, zl0 + BLK),
                   (zl1 - BLK, zl1)):
        adds.append(box(xa, xb, -BLK_P, 0.01, za, zb))

# crush ribs: small teeth at both rims of every channel
for sx in (1, -1):
    for sz in (1, -1):
        zg = Z_C + sz * G_DZ
        for rx in RIB_X:
            xr = sx * rx
            adds.append(box(xr - RIB_HW, xr + RIB_HW, 0, RIB_T,
                            zg + G_R - RIB_D, zg + G_R + 0.05))
            adds.append(box(xr - RIB_HW, xr + RIB_HW, 0, RIB_T,
                            zg - G_R - 0.05, zg - G_R + RIB_D))

# latch ears: D boss in front of the plate + round pip reaching into the pocket
hc = math.sqrt(EAR_R ** 2 - EAR_YC ** 2)      # half chord on the front face
windows = []
for sz in (1, -1):
    edge = Z_C + sz * P_OUT
    z0 = edge if sz > 0 else edge - EAR_OUT
    w0, w1 = sorted((edge - sz * WIN_Z1, edge - sz * WIN_Z0))
    for sx in (1, -1):
        xc = sx * EAR_X
        d = (cq.Workplane("XY", origin=(0, 0, z0))
             .moveTo(xc - hc, 0.02)
             .lineTo(xc - hc, 0)
             .threePointArc((xc, EAR_YC - EAR_R), (xc + hc, 0))
             .lineTo(xc + hc, 0.02)
             .close()
             .extrude(EAR_OUT).val())
        adds.append(d)
        adds.append(cq.Solid.makeCone(PIP_R0, PIP_R1, PIP_H + 0.01,
                                      pnt=cq.Vector(xc, EAR_YC, edge + sz * 0.01),
                                      dir=cq.Vector(0, 0, -sz)))
        windows.append(box(xc - WIN_W / 2, xc + WIN_W / 2, P_D, T + 1, w0, w1))

body = body.fuse(*adds).clean()

# ------------------------------------------------------------------ second set of cuts
cuts2 = list(windows)

# engraved marking
try:
    def glyph(ch, size, x_left, z_base):
        wp = cq.Workplane(cq.Plane(origin=(x_left, 0, z_base), xDir=(1, 0, 0),
                                   normal=(0, -1, 0)))
        return wp.text(ch, size, -TXT_DEPTH, combine=False, font=TXT_FONT,
                       halign="left", valign="bottom")

    for ch, size, xl, zb in TXT_GLYPHS:
        cuts2.extend(glyph(ch, size, xl, zb).solids().vals())
except Exception:
    pass

body = body.cut(*cuts2).clean()

result = cq.Workplane("XY").add(body)

VIEW = {"azimuth": 45, "elevation": 26}
